import cadquery as cq

# =====================================================================
#  Sheet-metal style mounting tray / frame
#  open top, bottom flange with a large rectangular opening,
#  inner ledge along the left, front and right walls,
#  hole rows, countersunk corner holes, keyhole slot, back-wall notches
# =====================================================================

# ---------------- overall size (mm) ----------------
W = 300.0           # length along X (front / back walls)
D = 238.0           # depth along Y (left / right walls)
H = 43.6            # wall height
T = 3.6             # wall thickness
TF = 1.8            # bottom flange thickness
OPEN_M = 25.5       # bottom opening inset from the outside on every side

# ---------------- inner ledge ----------------
LEDGE_SIDE = 12.8   # ledge inner face distance from outside (left / right)
LEDGE_FRONT = 14.5  # ledge inner face distance from outside (front)
LEDGE_Z = 14.5      # ledge top height
PLATE_T = 0.7       # thin doubler plates on the back wall at the two back corners

# ---------------- left wall slots / ledge notches ----------------
SLOT_L = 16.0                   # slot length along Y
SLOT_DEPTH = 5.3                # notch depth below the ledge top
SLOT_UP = 1.7                   # wall slot extends this much above the ledge top
SLOT_FRACS = (0.2, 0.4, 0.6, 0.8)  # slot centres as fraction of D

# ---------------- hole rows ----------------
HOLE_D = 6.5        # plain holes
HOLE_Z = H - 8.0    # hole row height
PITCH = 15.0        # hole pitch
N_SIDE = 8          # plain holes on each side of the keyhole (front wall)
CS_X = 11.5         # countersunk hole distance from the wall ends
CS_Z = H - 7.5      # countersunk hole height
CS_D = 5.5          # countersunk through diameter
CS_OD = 12.0        # countersink diameter (90 deg)

# ---------------- back wall ----------------
NOTCHES = ((63.0, 102.5), (138.0, 162.8))   # x-ranges from the left end
NOTCH_DEPTH = 20.6
BACK_HOLES = (30.0, 45.0, 120.0) + tuple(180.0 + PITCH * k for k in range(7))

# ---------------- keyhole slot (front wall centre) ----------------
KEY_W = 11.0
KEY_TOP = H - 3.8
KEY_BOT = H - 26.4
KEY_BUMP_R = 4.0
KEY_BUMP_Z = H - 14.7
KEY_CH_TOP = 3.5
KEY_CH_BOT = 4.5


def box(x0, x1, y0, y1, z0, z1):
    return cq.Solid.makeBox(x1 - x0, y1 - y0, z1 - z0,
                            pnt=cq.Vector(x0, y0, z0))


def ycyl(x, z, d, y0, y1):
    """cylinder along +Y from y0 to y1"""
    return cq.Solid.makeCylinder(d / 2.0, y1 - y0,
                                 pnt=cq.Vector(x, y0, z),
                                 dir=cq.Vector(0, 1, 0))


def cs_hole(x, z, y_face, inward):
    """through hole + 90 deg countersink opening at the outer face"""
    thru = ycyl(x, z, CS_D, -1.0, D + 1.0)
    cone = cq.Solid.makeCone(CS_OD / 2.0, 0.0, CS_OD / 2.0,
                             pnt=cq.Vector(x, y_face - inward * 0.01, z),
                             dir=cq.Vector(0, inward, 0))
    return [thru, cone]


# ---------------- tray: walls + bottom flange ----------------
tray = cq.Workplane("XY").add(box(0, W, 0, D, 0, H))
tray = tray.cut(box(T, W - T, T, D - T, TF, H + 1))
tray = tray.cut(box(OPEN_M, W - OPEN_M, OPEN_M, D - OPEN_M, -1, TF + 1))

# ---------------- inner ledge (U along left, front, right) ----------------
adds = [
    box(T, LEDGE_SIDE, T, D - T, 0, LEDGE_Z),                 # left
    box(W - LEDGE_SIDE, W - T, T, D - T, 0, LEDGE_Z),         # right
    box(T, W - T, T, LEDGE_FRONT, 0, LEDGE_Z),                # front
    box(T, LEDGE_SIDE, D - T - PLATE_T, D - T, 0, H),         # back-left doubler
    box(W - LEDGE_SIDE, W - T, D - T - PLATE_T, D - T, 0, H), # back-right doubler
]
body = tray.val().fuse(*adds).clean()

# ---------------- cutters ----------------
cuts = []

# left wall: slots through the wall + notches in the ledge
for f in SLOT_FRACS:
    yc = D * f
    cuts.append(box(-1, LEDGE_SIDE + 0.01, yc - SLOT_L / 2, yc + SLOT_L / 2,
                    LEDGE_Z - SLOT_DEPTH, LEDGE_Z + 0.01))
    cuts.append(box(-1, T + 0.01, yc - SLOT_L / 2, yc + SLOT_L / 2,
                    LEDGE_Z - SLOT_DEPTH, LEDGE_Z + SLOT_UP))

# back wall notches from the top edge
for (a, b) in NOTCHES:
    cuts.append(box(a, b, D - T - PLATE_T - 1, D + 1, H - NOTCH_DEPTH, H + 1))

# front wall hole row (symmetric about the keyhole)
cx = W / 2.0
for k in range(1, N_SIDE + 1):
    for s in (-1, 1):
        cuts.append(ycyl(cx + s * PITCH * k, HOLE_Z, HOLE_D, -1, T + 1))

# back wall holes
for x in BACK_HOLES:
    cuts.append(ycyl(x, HOLE_Z, HOLE_D, D - T - PLATE_T - 1, D + 1))

# countersunk corner holes, front and back
for x in (CS_X, W - CS_X):
    cuts += cs_hole(x, CS_Z, 0.0, 1)
    cuts += cs_hole(x, CS_Z, D, -1)

body = body.cut(*cuts)

# keyhole slot: chamfered slot with a round bump on the left edge
hw = KEY_W / 2.0
pts = [(-hw, KEY_TOP), (hw - KEY_CH_TOP, KEY_TOP), (hw, KEY_TOP - KEY_CH_TOP),
       (hw, KEY_BOT + KEY_CH_BOT), (hw - KEY_CH_BOT, KEY_BOT), (-hw, KEY_BOT)]
key = (cq.Workplane("XZ").workplane(offset=1.0)
       .polyline([(cx + u, v) for (u, v) in pts]).close()
       .extrude(-(LEDGE_FRONT + 2.0)))
bump = (cq.Workplane("XZ").workplane(offset=2.0)
        .center(cx - hw, KEY_BUMP_Z).circle(KEY_BUMP_R)
        .extrude(-(LEDGE_FRONT + 4.0)))
body = body.cut(key.cut(bump).val()).clean()

# centre the part on the origin in X/Y, sitting on z = 0
result = cq.Workplane("XY").add(body.translate(cq.Vector(-W / 2.0, -D / 2.0, 0)))

VIEW = {"azimuth": 45, "elevation": 26}
